import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# Drum housing, axis along +Y, front face at Y=0
R_CAP = 113.0        # front cap radius
L_CAP = 26.0         # front cap length
R_GROOVE = 90.0      # waist groove radius
Y_BODY = 80.0        # start of rear body
R_BODY = 110.0       # rear body radius
Y_FLANGE = 136.0     # start of rear flange
R_FLANGE = 117.5     # rear flange radius
Y_BACK = 147.0       # back face
F_CAP_FRONT = 1.0
F_SMALL = 2.0
F_CAP_BACK = 3.0
F_BODY_FRONT = 3.0
F_GROOVE = 5.0

# Right-angle gearbox, axis along +X at (Y=GB_Y, Z=0)
GB_Y = 45.0
R_NECK = 80.0
X_GB0 = 121.0        # back face of gearbox housing
R_GB = 99.0          # gearbox housing radius
X_BFL = 163.0        # start of bolt flange
R_BFL = 95.0
X_COVER = 177.0      # start of output cover
R_COVER = 79.8
X_END = 197.0        # output face

BOLT_PCD_R = 87.5
BOLT_HEAD_R = 6.7
BOLT_HEAD_H = 8.0
N_BOLTS = 8
SMALL_HOLE_R = 3.0

COVER_HOLE_R = 47.5  # pitch radius of the holes on the output face

# flat pads (two tapped holes) top & bottom of gearbox
PAD_X0, PAD_X1 = 112.0, 136.5
PAD_Z = 93.0
PAD_HALF_W = math.sqrt(R_GB ** 2 - PAD_Z ** 2)
PAD_HOLE_DY = 24.0

# slanted trim of the neck in front of the drum face
TRIM_P1 = (103.3, 0.0)
TRIM_P2 = (121.0, -32.0)

# side boss on -X side of the drum (rib over waist + body, square pad, plug)
BOSS_Z0, BOSS_Z1 = -1.0, 40.0
RIB_X_OUT = -111.5
RIB_Y0, RIB_Y1 = 26.0, 136.0
PAD_SQ_X_OUT = -120.5
PAD_SQ_Y0, PAD_SQ_Y1 = 29.0, 76.0
PLUG_R = 11.3
PLUG_Z = 20.8
PLUG_X_OUT = -122.5

# filler block between neck, rear flange and gearbox back face
FILL_X0 = 100.0
FILL_Y0, FILL_Y1 = 110.0, 140.5
FILL_Z = 29.0

# U-shaped notch at top of drum front cap
NOTCH_W = 10.4
NOTCH_D = 7.3
NOTCH_L = 14.0


def sel_circles(wp, pred):
    """select circular edges matching pred(radius, center)"""
    out = []
    for e in wp.edges().vals():
        if e.geomType() != "CIRCLE":
            continue
        if pred(e.radius(), e.Center()):
            out.append(e)
    return out


def fillet_where(wp, r, pred):
    edges = sel_circles(wp, pred)
    if not edges:
        return wp
    return wp.newObject(edges).fillet(r)


# ---------------- drum housing (revolved about Y) ----------------
prof = [
    (0, 0), (R_CAP, 0), (R_CAP, L_CAP), (R_GROOVE, L_CAP),
    (R_GROOVE, Y_BODY), (R_BODY, Y_BODY), (R_BODY, Y_FLANGE),
    (R_FLANGE, Y_FLANGE), (R_FLANGE, Y_BACK), (0, Y_BACK),
]
housing = (cq.Workplane("XY").polyline(prof).close()
           .revolve(360, (0, 0, 0), (0, 1, 0)))


def near(a, b, tol=0.5):
    return abs(a - b) < tol


housing = fillet_where(housing, F_CAP_FRONT,
                       lambda r, c: near(r, R_CAP) and near(c.y, 0))
housing = fillet_where(housing, F_CAP_BACK,
                       lambda r, c: near(r, R_CAP) and near(c.y, L_CAP))
housing = fillet_where(housing, F_GROOVE,
                       lambda r, c: near(r, R_GROOVE))
housing = fillet_where(housing, F_BODY_FRONT,
                       lambda r, c: near(r, R_BODY) and near(c.y, Y_BODY))
housing = fillet_where(housing, F_SMALL,
                       lambda r, c: near(r, R_BODY) and near(c.y, Y_FLANGE))
housing = fillet_where(housing, F_SMALL,
                       lambda r, c: near(r, R_FLANGE))

# U-notch at top of the front cap (round bottom, open at the rim)
NOTCH_ZC = R_CAP - NOTCH_D + NOTCH_W / 2
notch = (cq.Workplane("XZ", origin=(0, -1.0, NOTCH_ZC))
         .circle(NOTCH_W / 2).extrude(-(NOTCH_L + 1.0))
         .union(cq.Workplane("XZ", origin=(0, -1.0, NOTCH_ZC + 6.0))
                .rect(NOTCH_W, 12.0).extrude(-(NOTCH_L + 1.0))))
housing = housing.cut(notch)

# ---------------- neck ----------------
neck = (cq.Workplane("YZ", origin=(0, GB_Y, 0)).circle(R_NECK)
        .extrude(X_GB0 + 1))
sx = (TRIM_P2[0] - TRIM_P1[0]) / (TRIM_P2[1] - TRIM_P1[1])
cutter = (cq.Workplane("XY", origin=(0, 0, -200))
          .polyline([(-300, 0), TRIM_P1, TRIM_P2,
                     (TRIM_P1[0] + sx * (-300 - TRIM_P1[1]), -300),
                     (-300, -300)]).close()
          .extrude(400))
neck = neck.cut(cutter)

body = housing.union(neck)

# ---------------- gearbox (revolved about its X axis) ----------------
gprof = [
    (X_GB0, 0), (X_GB0, R_GB), (X_BFL, R_GB), (X_BFL, R_BFL),
    (X_COVER, R_BFL), (X_COVER, R_COVER), (X_END, R_COVER), (X_END, 0),
]
gb = (cq.Workplane("XY", origin=(0, GB_Y, 0)).polyline(gprof).close()
      .revolve(360, (0, 0, 0), (1, 0, 0)))
gb = fillet_where(gb, 2.5, lambda r, c: near(r, R_GB) and near(c.x, X_BFL))
gb = fillet_where(gb, 3.0, lambda r, c: near(r, R_COVER) and near(c.x, X_END))
gb = fillet_where(gb, 1.0, lambda r, c: near(r, R_BFL) and near(c.x, X_COVER))

# flats top and bottom plus pad blocks reaching back over the neck
for s in (1, -1):
    flat_cut = (cq.Workplane("XY")
                .box(PAD_X1 - X_GB0 + 1, 2 * R_GB + 10, 20,
                     centered=(False, True, False))
                .translate((X_GB0 - 1, GB_Y, PAD_Z)))
    if s < 0:
        flat_cut = flat_cut.mirror("XY")
    gb = gb.cut(flat_cut)

body = body.union(gb)

for s in (1, -1):
    pad = (cq.Workplane("XY")
           .box(X_GB0 - PAD_X0 + 1, 2 * PAD_HALF_W, 25,
                centered=(False, True, False))
           .edges("|Z").edges("<X").fillet(4.0)
           .translate((PAD_X0, GB_Y, PAD_Z - 25)))
    if s < 0:
        pad = pad.mirror("XY")
    body = body.union(pad)
    # two counterbored holes on each pad
    for dy in (-PAD_HOLE_DY, PAD_HOLE_DY):
        hole = (cq.Workplane("XY", origin=(X_GB0, GB_Y + dy, s * PAD_Z))
                .circle(3.0).extrude(-s * 14))
        cb = (cq.Workplane("XY", origin=(X_GB0, GB_Y + dy, s * PAD_Z))
              .circle(5.0).extrude(-s * 1.5))
        body = body.cut(hole).cut(cb)

# ---------------- bolts, holes on the output side ----------------
for i in range(N_BOLTS):
    a = math.radians(360.0 / N_BOLTS * i)
    y = GB_Y + BOLT_PCD_R * math.cos(a)
    z = BOLT_PCD_R * math.sin(a)
    head = (cq.Workplane("YZ", origin=(X_COVER - 0.2, y, z))
            .circle(BOLT_HEAD_R).extrude(BOLT_HEAD_H + 0.2))
    head = head.faces(">X").edges().fillet(0.8)
    body = body.union(head)

for i in range(4):
    a = math.radians(22.5 + 90 * i)
    y = GB_Y + BOLT_PCD_R * math.cos(a)
    z = BOLT_PCD_R * math.sin(a)
    body = body.cut(cq.Workplane("YZ", origin=(X_COVER + 0.5, y, z))
                    .circle(SMALL_HOLE_R).extrude(-10))

# holes on the output face: (angle deg, radius)
COVER_HOLES = [(45, 6.5), (135, 6.5), (180, 7.6), (225, 6.5), (315, 6.5),
               (-15.5, 6.5), (90, 3.5), (270, 3.5)]
for ang, hr in COVER_HOLES:
    a = math.radians(ang)
    y = GB_Y + COVER_HOLE_R * math.cos(a)
    z = COVER_HOLE_R * math.sin(a)
    body = body.cut(cq.Workplane("YZ", origin=(X_END + 1, y, z))
                    .circle(hr).extrude(-13))

# ---------------- side boss on the drum ----------------
rib = (cq.Workplane("XY")
       .box(-80.0 - RIB_X_OUT, RIB_Y1 - RIB_Y0, BOSS_Z1 - BOSS_Z0,
            centered=False)
       .translate((RIB_X_OUT, RIB_Y0, BOSS_Z0)))
body = body.union(rib)
sq = (cq.Workplane("XY")
      .box(RIB_X_OUT - PAD_SQ_X_OUT + 1.0, PAD_SQ_Y1 - PAD_SQ_Y0, BOSS_Z1 - BOSS_Z0,
           centered=False)
      .edges("<X and >Z").chamfer(4.0)
      .edges("<X and (<Y or >Y or <Z)").chamfer(1.2)
      .translate((PAD_SQ_X_OUT, PAD_SQ_Y0, BOSS_Z0)))
body = body.union(sq)
plug = (cq.Workplane("YZ", origin=(PAD_SQ_X_OUT + 0.5, (PAD_SQ_Y0 + PAD_SQ_Y1) / 2,
                                   PLUG_Z))
        .circle(PLUG_R).extrude(-(PAD_SQ_X_OUT + 0.5 - PLUG_X_OUT)))
plug = plug.faces("<X").edges().chamfer(0.8)
body = body.union(plug)

# filler block at the rear side of the neck
fill = (cq.Workplane("XY")
        .box(X_GB0 + 0.5 - FILL_X0, FILL_Y1 - FILL_Y0, 2 * FILL_Z, centered=False)
        .translate((FILL_X0, FILL_Y0, -FILL_Z)))
body = body.union(fill)

# two axial index marks on the bolt flange rim
for dy in (-5.0, -13.0):
    zs = math.sqrt(R_BFL ** 2 - dy ** 2) - 0.8
    mark = (cq.Workplane("XY", origin=(X_BFL + 7.0, GB_Y + dy, zs))
            .rect(10.0, 0.8).extrude(5))
    body = body.cut(mark)

result = body
